import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
TUBE_OD = 50.0          # tube outer diameter
TUBE_ID = 39.2          # tube bore
TUBE_LEN = 82.5         # tube length
TUBE_YAW = 11.0         # tube axis rotated from +Y towards +X (deg, about Z)
BOLT_AXIAL = 4.7        # bolt position along the tube axis from tube centre (towards +Y end)
BOLT_LATERAL = 1.3      # bolt offset sideways from the tube axis (towards +X)

BOLT_D = 19.3           # bolt shank diameter
NUT_AF = 25.45          # across flats of nut and bolt head
NUT_H = 12.2            # nut height
HEAD_H = 12.3           # bolt head height
GAP_TOP = 1.0           # clearance between nut and tube surface
GAP_BOT = 2.3           # clearance between bolt head and tube surface
CHAMFER_ANG = 30.0      # nut / head corner chamfer angle
CHAMFER_DIA = 0.95      # chamfer circle as fraction of across flats
BOLT_PROTRUDE = 0.8     # bolt end sticking out above the nut
BOLT_END_CH = 1.3       # radial size of the chamfer on the bolt end
HEAD_FILLET = 1.0       # fillet under the bolt head

VIEW = {"azimuth": 45, "elevation": 26}

# cosmetic: angular position of the seams of the revolved / cylindrical faces
SEAM_ANG = 135.0        # bolt, nut and head seams (deg about Z, towards the back)
TUBE_SEAM_OUT = 234.5   # outer tube seam, deg about the tube axis from the +X side
TUBE_SEAM_IN = 54.5     # bore seam

R = TUBE_OD / 2.0


def hex_prism(af, h, z0, top_ch=True, bot_ch=True):
    """Hex prism with corners on +/-X, from z0 to z0+h, with conical corner chamfers."""
    ac = af / math.cos(math.radians(30))
    body = (cq.Workplane("XY").workplane(offset=z0)
            .polygon(6, ac).extrude(h))
    rc = CHAMFER_DIA * af / 2.0
    t = math.tan(math.radians(CHAMFER_ANG))
    rbig = ac / 2.0 + 2.0
    dz = (rbig - rc) * t
    pts = [(0, z0 - 1)]
    if bot_ch:
        pts += [(0, z0), (rc, z0), (rbig, z0 + dz)]
    else:
        pts += [(rbig, z0 - 1)]
    if top_ch:
        pts += [(rbig, z0 + h - dz), (rc, z0 + h), (0, z0 + h)]
    else:
        pts += [(rbig, z0 + h + 1), (0, z0 + h + 1)]
    # remove duplicate leading point when the bottom is chamfered
    if bot_ch:
        pts = pts[1:]
    keep = (cq.Workplane("XZ").polyline(pts).close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
            .rotate((0, 0, 0), (0, 0, 1), SEAM_ANG))
    return body.intersect(keep)


# ---------------- tube (axis along Y, then yawed) ----------------
# seams of the outer / inner cylinders are turned to where they are least visible
so, si = math.radians(TUBE_SEAM_OUT), math.radians(TUBE_SEAM_IN)
outer = (cq.Workplane(cq.Plane(origin=(0, -TUBE_LEN / 2.0, 0),
                               xDir=(math.cos(so), 0, math.sin(so)), normal=(0, 1, 0)))
         .circle(R).extrude(TUBE_LEN))
bore = (cq.Workplane(cq.Plane(origin=(0, -TUBE_LEN / 2.0 - 1, 0),
                              xDir=(math.cos(si), 0, math.sin(si)), normal=(0, 1, 0)))
        .circle(TUBE_ID / 2.0).extrude(TUBE_LEN + 2))
tube = outer.cut(bore)
# put the bolt axis at the origin
tube = tube.translate((-BOLT_LATERAL, -BOLT_AXIAL, 0))
tube = tube.rotate((0, 0, 0), (0, 0, 1), -TUBE_YAW)

# ---------------- bolt ----------------
z_nut0 = R + GAP_TOP
z_nut1 = z_nut0 + NUT_H
z_head1 = -(R + GAP_BOT)
z_head0 = z_head1 - HEAD_H
z_end = z_nut1 + BOLT_PROTRUDE
rb = BOLT_D / 2.0

shank = (cq.Workplane("XZ")
         .polyline([(0, z_head0 + 1), (rb, z_head0 + 1), (rb, z_nut1),
                    (rb - BOLT_END_CH, z_end), (0, z_end)]).close()
         .revolve(360, (0, 0, 0), (0, 1, 0))
         .rotate((0, 0, 0), (0, 0, 1), SEAM_ANG))

nut = hex_prism(NUT_AF, NUT_H, z_nut0)
head = hex_prism(NUT_AF, HEAD_H, z_head0)

# bolt = shank + head, with a fillet where the shank leaves the head
bolt = shank.union(head).val()
under_head = [e for e in bolt.Edges()
              if e.geomType() == "CIRCLE"
              and abs(e.radius() - rb) < 1e-3
              and abs(e.Center().z - z_head1) < 1e-3]
bolt = bolt.fillet(HEAD_FILLET, under_head)

result = tube.union(cq.Workplane("XY").add(bolt)).union(nut)
